import math
import cadquery as cq
from OCP.BRepOffsetAPI import BRepOffsetAPI_ThruSections
from OCP.GeomAbs import GeomAbs_C1

# ---------------- driving dimensions (mm) ----------------
# Organic kidney shaped knob: a domed kidney-shaped head that tapers down
# into an offset tail; the +Y side is trimmed by a large smooth face.

PTS_PER_QUAD = 6   # spline points per quadrant arc of a loft section
SEAM_SHIFT = 1     # start point offset of the section splines
LOFT_SMOOTHING = False
LOFT_MAX_DEGREE = 3

# Horizontal loft sections.  Each section is four superellipse quadrant arcs
# joining its four extreme points:
#   z,
#   (xmin, y at xmin), (xmax, y at xmax), (ymin, x at ymin), (ymax, x at ymax),
#   exponents of quadrants (+X+Y, -X+Y, -X-Y, +X-Y),
#   kidney notch on the -X side (depth, centre offset towards +Y, half-width)
SECTIONS = [
    (1.2, (5.2, -15.0), (10.8, -13.4), (-16.9, 6.5), (-12.5, 8.0),
     (2.2, 1.6, 2.0, 2.1), (0.0, 0.0, 0.8)),
    (4.5, (4.7, -13.0), (13.9, -10.5), (-16.1, 5.5), (-6.9, 9.0),
     (2.2, 2.4, 2.4, 1.5), (0.0, 0.0, 0.8)),
    (10.0, (4.2, -8.4), (15.6, -6.6), (-15.4, 5.6), (0.0, 9.0),
     (2.2, 1.9, 2.0, 1.7), (0.0, 0.0, 0.8)),
    (17.0, (1.0, -3.8), (15.7, -1.0), (-18.0, 2.5), (6.4, 8.0),
     (2.8, 2.1, 2.0, 1.6), (0.0, 0.0, 0.8)),
    (20.5, (-8.2, -7.6), (15.7, 1.3), (-20.0, -1.6), (9.0, 6.5),
     (2.9, 2.0, 2.0, 1.8), (5.0, 0.0, 0.6)),
    (24.0, (-11.4, -7.5), (15.6, 3.6), (-20.0, -4.9), (12.0, 5.0),
     (3.0, 2.0, 2.3, 2.2), (6.3, 0.0, 0.6)),
    (31.0, (-16.1, -3.2), (13.9, 5.8), (-17.6, -7.2), (17.6, 0.8),
     (2.6, 2.2, 3.0, 2.2), (5.5, 0.0, 0.7)),
    (38.0, (-15.3, 0.6), (11.6, 9.0), (-12.9, -4.2), (20.6, -1.4),
     (1.7, 2.0, 2.5, 1.8), (4.5, 0.0, 0.8)),
    (44.0, (-12.5, 10.1), (5.0, 10.8), (-5.2, -4.2), (18.2, -2.4),
     (2.4, 2.2, 1.6, 2.2), (0.5, 0.0, 0.8)),
    (47.6, (-10.4, 9.0), (1.3, 10.6), (1.6, -5.4), (15.2, -4.0),
     (1.8, 1.8, 2.0, 2.0), (0.0, 0.0, 0.8)),
    (49.3, (-8.5, 9.0), (-2.9, 9.0), (5.8, -5.8), (12.2, -5.6),
     (2.0, 2.0, 2.0, 2.0), (0.0, 0.0, 0.8)),
    (49.85, (-6.7, 9.0), (-4.5, 9.0), (7.7, -5.8), (10.3, -5.8),
     (2.0, 2.0, 2.0, 2.0), (0.0, 0.0, 0.8)),
]
TIP_R = 1.3                      # radius of the small flat end of the tail
TIP_BOTTOM = (7.9, -15.0, 0.0)   # centre of the tail's end
TIP_TOP = (-5.8, 9.0, 50.0)      # apex of the dome

# profile (Y, Z) of the large trimming face on the +Y side (seen from +X)
TRIM_PROFILE = [
    (-16.5, -1.0), (-13.2, 1.0), (-11.1, 2.8), (-8.4, 5.0), (-4.7, 8.1),
    (-1.1, 11.8), (1.1, 14.5), (3.7, 18.1), (6.3, 21.3), (9.0, 24.2),
    (12.1, 27.7), (14.0, 29.9), (15.3, 32.5), (17.4, 36.2), (19.3, 39.6),
    (21.0, 43.0), (23.5, 50.0), (26.0, 56.0),
]


def section_wire(z, pxmin, pxmax, pymin, pymax, quad_n, notch):
    x0, yx0 = pxmin
    x1, yx1 = pxmax
    y0, xy0 = pymin
    y1, xy1 = pymax
    depth, centre, width = notch
    # quadrant arcs in CCW order starting at +Y extreme:
    # (centre x, centre y, semi x, semi y, sign x, sign y, exponent)
    arcs = [
        (xy1, yx0, xy1 - x0, y1 - yx0, -1, +1, quad_n[1]),  # -X+Y
        (xy0, yx0, xy0 - x0, yx0 - y0, -1, -1, quad_n[2]),  # -X-Y
        (xy0, yx1, x1 - xy0, yx1 - y0, +1, -1, quad_n[3]),  # +X-Y
        (xy1, yx1, x1 - xy1, y1 - yx1, +1, +1, quad_n[0]),  # +X+Y
    ]
    pts = []
    for k, (cx, cy, ax, ay, sx, sy, n) in enumerate(arcs):
        e = 2.0 / n
        for j in range(PTS_PER_QUAD):
            a = 0.5 * math.pi * j / PTS_PER_QUAD
            # walk from the "vertical" extreme to the "horizontal" extreme
            if k in (0, 2):
                u, v = math.sin(a) ** e, math.cos(a) ** e
            else:
                u, v = math.cos(a) ** e, math.sin(a) ** e
            x = cx + sx * ax * u
            y = cy + sy * ay * v
            if sx < 0 and depth > 0:  # kidney notch in the -X side
                t = (sy * v - centre) / width
                x += depth * max(0.0, 1.0 - t * t) ** 2 * u
            pts.append(cq.Vector(x, y, z))
    pts = pts[SEAM_SHIFT:] + pts[:SEAM_SHIFT]   # loft seam just off the +Y extreme
    # uniform parameters keep corresponding points of all sections aligned
    params = [i / len(pts) for i in range(len(pts) + 1)]
    edge = cq.Edge.makeSpline(pts, periodic=True, parameters=params)
    return cq.Wire.assembleEdges([edge])


def smooth_loft(wires, apex):
    """Loft through the section wires, closing the top in a single apex."""
    builder = BRepOffsetAPI_ThruSections(True, False, 1e-6)
    builder.SetSmoothing(LOFT_SMOOTHING)
    builder.SetMaxDegree(LOFT_MAX_DEGREE)
    builder.SetContinuity(GeomAbs_C1)
    builder.CheckCompatibility(True)
    for w in wires:
        builder.AddWire(w.wrapped)
    builder.AddVertex(cq.Vertex.makeVertex(*apex).wrapped)
    builder.Build()
    return cq.Solid(builder.Shape())


def tip_section(p):
    x, y, z = p
    return (z, (x - TIP_R, y), (x + TIP_R, y), (y - TIP_R, x), (y + TIP_R, x),
            (2.0, 2.0, 2.0, 2.0), (0.0, 0.0, 0.8))


wires = [section_wire(*s) for s in [tip_section(TIP_BOTTOM)] + SECTIONS]
body = cq.Workplane("XY").add(smooth_loft(wires, TIP_TOP))

# region kept: everything on the -Y side of the trimming profile
y0, z0 = TRIM_PROFILE[0]
y1, z1 = TRIM_PROFILE[-1]
keeper = (
    cq.Workplane("YZ", origin=(-40, 0, 0))
    .moveTo(y0, z0)
    .spline(TRIM_PROFILE[1:], includeCurrent=True)
    .lineTo(-60, z1)
    .lineTo(-60, z0 - 10)
    .lineTo(y0, z0 - 10)
    .close()
    .extrude(80)
)
result = body.intersect(keeper)

VIEW = {"azimuth": 45, "elevation": 26}
